import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PITCH = 10.0          # fin / slot pitch
N_PITCH = 24          # plate length in pitches
L = PITCH * N_PITCH   # plate length (X)
H = 70.0              # plate height (Z)
T_BASE = 6.2          # base plate thickness (Y) = groove floor
T_TOP = 7.5           # overall depth at the top (fin tips)
T_BOT = 16.0          # overall depth at the bottom (fin tips)
CORNER_R = 5.0        # plate outline corner radius (XZ)

GROOVE_W = 5.7        # gap between fins
FIN_TIP_R = 0.8       # rounding of fin tip edges

SLOT_W = GROOVE_W     # vent slot width (opens exactly into the groove behind)
SLOT_LEN = 26.0       # vent slot length
SLOT_MARGIN = 6.1     # slot distance from top / bottom edge
SLOT_POS = [1, 2, 3, 4, 5, 7, 8, 9, 10, 11, 12, 17, 18, 19, 21, 22, 23]

BOSS_X = [60.3, 200.9]  # boss centres from the left edge; first one is keyed
BOSS_Z = 16.2         # boss centre height from the bottom
BOSS_D = 11.8
BOSS_H = 5.4          # boss protrusion from the front face
BOSS_HOLE_D = 6.6
BOSS_HOLE_DEPTH = 8.0
KEY_FLAT = 4.9        # keyed boss: left / bottom flats at this distance from centre
KEY_FILLET = 1.2      # corner rounding of the keyed boss' squared corner

PAD_XC = 144.6       # pad centre (from left edge)
PAD_W = 30.0
PAD_H = 20.4
PAD_ZC = H - 24.0
PAD_T = 3.0

RECESS_X0 = 5 * PITCH  # recess under the keyed boss (from left edge)
RECESS_X1 = 7 * PITCH
RECESS_TOP = BOSS_Z - KEY_FLAT
RECESS_DEPTH = 1.5


def xpos(i):
    """X coordinate of pitch index i (part centred on X=0)."""
    return -L / 2.0 + i * PITCH


def yslant(z):
    """Y of the fin-tip plane at height z."""
    return T_BOT + (T_TOP - T_BOT) * z / H


# ---------------- wedge body (side profile extruded along X) ----------------
# Y = 0 is the front face (slots), +Y is the finned back, Z up.
profile = (
    cq.Workplane("YZ", origin=(-L / 2.0, 0, 0))
    .polyline([(0, 0), (T_BOT, 0), (T_TOP, H), (0, H)])
    .close()
    .extrude(L)
)
body = profile.edges("|Y").fillet(CORNER_R)

# ---------------- fins: cut grooves into the back ----------------
grooves = None
for k in range(1, N_PITCH):
    g = (
        cq.Workplane("XY")
        .box(GROOVE_W, 40.0, H + 2.0, centered=(True, False, False))
        .translate((xpos(k), T_BASE, -1.0))
    )
    grooves = g if grooves is None else grooves.union(g)
body = body.cut(grooves)

# round the tip edges of every fin (edges in the slanted tip plane, except at the top)
tip_edges = []
for e in body.edges().vals():
    pts = (e.startPoint(), e.endPoint(), e.positionAt(0.5))
    on_tip = all(abs(p.y - yslant(p.z)) < 1e-3 for p in pts)
    at_top = all(abs(p.z - H) < 1e-3 for p in pts)
    if on_tip and not at_top:
        tip_edges.append(e)
body = cq.Workplane("XY").newObject([body.val().fillet(FIN_TIP_R, tip_edges)])

# ---------------- vent slots (through) ----------------
z_up = H - SLOT_MARGIN - SLOT_LEN / 2.0
z_lo = SLOT_MARGIN + SLOT_LEN / 2.0
slot_pts = []
for i in SLOT_POS:
    slot_pts.append((xpos(i), z_up))
    slot_pts.append((xpos(i), z_lo))
slots = (
    cq.Workplane("XZ", origin=(0, -1.0, 0))
    .pushPoints(slot_pts)
    .slot2D(SLOT_LEN, SLOT_W, angle=90)
    .extrude(-40.0)
)
body = body.cut(slots)

# ---------------- raised rectangular pad ----------------
pad = (
    cq.Workplane("XZ")
    .center(-L / 2.0 + PAD_XC, PAD_ZC)
    .rect(PAD_W, PAD_H)
    .extrude(PAD_T)
)
body = body.union(pad)

# ---------------- recess at the bottom edge below the keyed boss ----------------
recess = (
    cq.Workplane("XY")
    .box(RECESS_X1 - RECESS_X0, RECESS_DEPTH + 1.0, RECESS_TOP + 1.0, centered=False)
    .translate((xpos(0) + RECESS_X0, -1.0, -1.0))
)
body = body.cut(recess)

# ---------------- bosses with holes ----------------
r = BOSS_D / 2.0
k = KEY_FLAT
f = KEY_FILLET
c = (r * r - k * k) ** 0.5          # half chord where a flat meets the circle
for n, bx in enumerate(BOSS_X):
    cx, cz = -L / 2.0 + bx, BOSS_Z
    if n == 0:
        # keyed boss: round, with flats on the left and bottom meeting in a
        # (slightly rounded) square corner at the lower left
        boss = (
            cq.Workplane("XZ")
            .moveTo(cx + c, cz - k)
            .lineTo(cx - k + f, cz - k)
            .threePointArc((cx - k + f - f * 0.70711, cz - k + f - f * 0.70711),
                           (cx - k, cz - k + f))
            .lineTo(cx - k, cz + c)
            .threePointArc((cx + r * 0.70711, cz + r * 0.70711), (cx + c, cz - k))
            .close()
            .extrude(BOSS_H)
        )
    else:
        # plain round boss (seam turned to the hidden -X side)
        boss = (
            cq.Workplane("XZ")
            .circle(r)
            .extrude(BOSS_H)
            .rotate((0, 0, 0), (0, 1, 0), 180)
            .translate((cx, 0, cz))
        )
    body = body.union(boss)
    hole = (
        cq.Workplane("XZ", origin=(0, -BOSS_H, 0))
        .center(cx, cz)
        .circle(BOSS_HOLE_D / 2.0)
        .extrude(-BOSS_HOLE_DEPTH)
    )
    body = body.cut(hole)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
